import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_L = 85.0        # along X
PLATE_W = 60.0        # along Y
PLATE_T = 2.7         # thickness
CORNER_R = 3.0        # vertical corner radius

# leg / counterbore positions
LEG_X = (-36.3, 17.7)
LEG_Y = (-22.8, 22.8)
CB_D = 5.7            # counterbore diameter (top side)
CB_DEPTH = 1.85

LEG_D = 4.6
LEG_L = 19.2          # below plate underside
CONE_D = 8.8          # conical flare diameter at plate underside
CONE_H = 2.2
LEG_TIP_R = 0.45
LEG_HOLE_D = 3.0
LEG_HOLE_DEPTH = 6.0

# vent slots
SLOT_N = 9
SLOT_PITCH = 5.12
SLOT_X0 = -29.24
SLOT_W = 2.9
SLOT_LEN = 21.5
SLOT_ROW_Y = (13.5, -13.5)

# logo (octopus engraving)
LOGO_CX = 27.9
LOGO_CY = -0.4
LOGO_DEPTH = 0.8

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .box(PLATE_L, PLATE_W, PLATE_T, centered=(True, True, False))
    .edges("|Z")
    .fillet(CORNER_R)
)

# slots
slot_pts = []
for ry in SLOT_ROW_Y:
    for i in range(SLOT_N):
        slot_pts.append((SLOT_X0 + i * SLOT_PITCH, ry))
slots = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(slot_pts)
    .slot2D(SLOT_LEN, SLOT_W, angle=90)
    .extrude(PLATE_T + 2.0)
)
plate = plate.cut(slots)

# counterbores from the top
leg_pts = [(x, y) for x in LEG_X for y in LEG_Y]
cbs = (
    cq.Workplane("XY")
    .workplane(offset=PLATE_T - CB_DEPTH)
    .pushPoints(leg_pts)
    .circle(CB_D / 2.0)
    .extrude(CB_DEPTH + 1.0)
)
plate = plate.cut(cbs)

# ---------------- legs ----------------
r = LEG_D / 2.0
rc = CONE_D / 2.0
profile = [
    (0.0, -LEG_L),
    (r, -LEG_L),
    (r, -CONE_H),
    (rc, 0.0),
    (rc, 0.5),
    (0.0, 0.5),
]
leg_proto = (
    cq.Workplane("XZ").polyline(profile).close().revolve(360, (0, 0, 0), (0, 1, 0))
    .faces("<Z").edges().fillet(LEG_TIP_R)
)
leg_hole = (
    cq.Workplane("XY")
    .workplane(offset=-LEG_L - 0.5)
    .circle(LEG_HOLE_D / 2.0)
    .extrude(LEG_HOLE_DEPTH + 0.5)
)
leg_proto = leg_proto.cut(leg_hole)
# turn the revolve seam towards the back-left so it stays out of sight
leg_proto = leg_proto.rotate((0, 0, 0), (0, 0, 1), 135)

for (x, y) in leg_pts:
    plate = plate.union(leg_proto.translate((x, y, 0)))

# ---------------- octopus logo pocket ----------------
def wp_at(depth):
    return cq.Workplane("XY").workplane(offset=PLATE_T - depth).center(LOGO_CX, LOGO_CY)


def mirror_u(pts):
    return [(-u, v) for (u, v) in pts]


NECK_V = 0.94  # line where the head pocket meets the lower tentacles

# head: dome, eye surrounds and neck (depth LOGO_DEPTH)
D1 = LOGO_DEPTH
H1 = D1 + 1.0
head = wp_at(D1).center(0, 6.2).ellipse(4.0, 3.5).extrude(H1)
for s in (-1, 1):
    head = head.union(wp_at(D1).center(s * 3.15, 6.5).circle(2.4).extrude(H1))
neck_pts = [(-5.2, 5.6), (-4.1, 3.26), (-3.62, 2.05), (-3.6, NECK_V),
            (3.6, NECK_V), (3.62, 2.05), (4.1, 3.26), (5.2, 5.6)]
head = head.union(wp_at(D1).polyline(neck_pts).close().extrude(H1))

# upper tentacles: arching out of the neck and curling down to a point
up_outer = [(-5.56, 3.99), (-7.49, 5.43), (-8.94, 5.68), (-10.39, 5.19), (-11.35, 4.23),
            (-11.7, 2.78), (-11.65, 1.3)]
up_inner = [(-10.87, 2.78), (-9.9, 3.74), (-9.3, 3.86), (-8.45, 3.62), (-7.97, 3.02),
            (-7.6, 2.05), (-7.49, NECK_V)]


def upper_tentacle(outer, inner, base_start, base_end):
    w = (wp_at(D1).moveTo(*base_start)
         .spline(outer, includeCurrent=True)
         .spline(inner, includeCurrent=True)
         .lineTo(*base_end)
         .close())
    return w.extrude(H1)


head = head.union(upper_tentacle(up_outer, up_inner, (-3.62, 2.05), (-3.6, NECK_V)))
head = head.union(upper_tentacle(mirror_u(up_outer), mirror_u(up_inner), (3.62, 2.05), (3.6, NECK_V)))

# eyes stay raised: horseshoe islands inside the head pocket
for s in (-1, 1):
    eye = wp_at(D1).center(s * 3.15, 6.5).circle(2.1).extrude(H1)
    pupil = wp_at(D1).center(s * 2.95, 5.7).circle(0.95).extrude(H1)
    pupil_gap = wp_at(D1).center(s * 2.95, 4.6).rect(1.3, 2.2).extrude(H1)
    head = head.cut(eye.cut(pupil).cut(pupil_gap))

# lower tentacles (slightly deeper): wavy outer edge, zig-zag inner edge, curled tips
D2 = LOGO_DEPTH + 0.15
H2 = D2 + 1.0
zig_L = [(-1.45, NECK_V), (-1.45, 0.7), (-3.62, -0.87), (-1.69, -1.47), (-4.35, -2.56),
         (-1.45, -3.65), (-4.1, -4.0)]
inner_L = [(-3.99, -4.86), (-3.38, -6.18), (-4.23, -7.39), (-3.86, -8.3), (-2.6, -8.5), (-1.93, -8.36)]
lobe3_L = [(-2.75, -9.1), (-4.1, -9.45), (-5.4, -9.0), (-6.2, -7.7), (-6.25, -6.6), (-5.75, -5.65)]
lobe2_L = [(-7.0, -5.0), (-7.6, -3.9), (-7.3, -2.95), (-6.65, -2.45)]
lobe1_L = [(-7.4, -1.9), (-8.0, -0.4), (-7.73, NECK_V)]


def lower_tentacle(zig, inner, l3, l2, l1):
    w = wp_at(D2).moveTo(*zig[0])
    for p in zig[1:]:
        w = w.lineTo(*p)
    w = w.spline(inner, includeCurrent=True)
    w = w.spline(l3, includeCurrent=True)
    w = w.spline(l2, includeCurrent=True)
    w = w.spline(l1, includeCurrent=True)
    return w.close().extrude(H2)


lower = lower_tentacle(zig_L, inner_L, lobe3_L, lobe2_L, lobe1_L)
# the right-hand tentacle is not an exact mirror at its zig-zag edge
zig_R = [(0.72, NECK_V), (3.86, -1.11), (1.57, -0.87), (3.74, -2.32), (1.21, -3.65), (4.1, -4.0)]
lower = lower.union(lower_tentacle(zig_R, *[mirror_u(p) for p in (inner_L, lobe3_L, lobe2_L, lobe1_L)]))

plate = plate.cut(head).cut(lower)

result = plate
